import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_ARC = 50.0        # radius of each of the four eccentric lobe arcs
ECC = 7.75          # eccentricity of the lobe arcs (= lobe step height, roughly)
T = 20.7            # overall thickness (along Y)
R_CAV = 40.0        # radius of the front cylindrical recess
FLOOR = 1.53        # thickness of the perforated floor under the recess
PITCH = 3.92        # honeycomb cell pitch (centre to centre)
HEX_W = 3.05        # hex cell width across flats
HEX_BELOW = 1.38    # how far the hex cells run below the recess floor
HOLE_D = 3.56       # shallow round counterbore on the back face under every cell
EDGE_MARGIN = 0.88  # minimum wall between a cell and the outer contour
LAND_R = 2.8        # solid central land radius
CENTER_HOLE_D = 1.6   # centre through hole in the land

D_CAV = T - FLOOR               # recess depth
D_HEX = D_CAV + HEX_BELOW       # hex cell depth from the front face
Y_FRONT = -T / 2.0              # open (recessed) face, towards the front camera
Y_BACK = T / 2.0                # flat perforated back face
R_HEX = HEX_W / math.sqrt(3.0)  # circumradius of a hex cell
R_SMALL = R_ARC - ECC
R_BIG = math.sqrt(R_ARC ** 2 - ECC ** 2)
AXIS = cq.Vector(0, 1, 0)
# the back-skin hole must enclose the hex cell so the two layers nest cleanly
HOLE_R = max(HOLE_D, 2.0 * R_HEX + 0.02) / 2.0


def arc_center(k):
    a = math.radians(90.0 * k)
    return (-ECC * math.cos(a), -ECC * math.sin(a))


def polar(r, deg):
    a = math.radians(deg)
    return (r * math.cos(a), r * math.sin(a))


def outline_r(theta_deg):
    """radius of the ratchet contour at polar angle theta (front view, X right, Z up)"""
    k = int((theta_deg % 360.0) // 90.0)
    cx, cz = arc_center(k)
    ux, uz = math.cos(math.radians(theta_deg)), math.sin(math.radians(theta_deg))
    b = ux * cx + uz * cz
    return b + math.sqrt(b * b - (cx * cx + cz * cz) + R_ARC ** 2)


def seg_dist(p, a, b):
    dx, dz = b[0] - a[0], b[1] - a[1]
    t = ((p[0] - a[0]) * dx + (p[1] - a[1]) * dz) / (dx * dx + dz * dz)
    t = max(0.0, min(1.0, t))
    return math.hypot(p[0] - a[0] - t * dx, p[1] - a[1] - t * dz)


def boundary_dist(p):
    """distance from p to the ratchet contour (4 arcs + 4 radial steps)"""
    best = 1e9
    for k in range(4):
        cx, cz = arc_center(k)
        vx, vz = p[0] - cx, p[1] - cz
        L = math.hypot(vx, vz)
        qx, qz = cx + vx / L * R_ARC, cz + vz / L * R_ARC
        th = math.degrees(math.atan2(qz, qx)) % 360.0
        if 90.0 * k <= th <= 90.0 * (k + 1):
            best = min(best, abs(R_ARC - L))
        best = min(best, seg_dist(p, polar(R_SMALL, 90.0 * k), polar(R_BIG, 90.0 * k)))
    return best


def inside_outline(p):
    th = math.degrees(math.atan2(p[1], p[0])) % 360.0
    return math.hypot(*p) <= outline_r(th)


def outline_wire(y):
    """four-lobed ratchet contour in the XZ plane at height y"""
    w = cq.Workplane("XZ", origin=(0, y, 0)).moveTo(*polar(R_SMALL, 0.0))
    for k in range(4):
        cx, cz = arc_center(k)
        ex, ez = polar(R_BIG, 90.0 * (k + 1))
        f0 = 90.0 * k
        f1 = math.degrees(math.atan2(ez - cz, ex - cx))
        if f1 < f0:
            f1 += 360.0
        fm = math.radians(0.5 * (f0 + f1))
        w = w.threePointArc((cx + R_ARC * math.cos(fm), cz + R_ARC * math.sin(fm)), (ex, ez))
        if k < 3:
            w = w.lineTo(*polar(R_SMALL, 90.0 * (k + 1)))
    return w.close().wires().val()


def hex_wire(x, z, y):
    vs = [
        cq.Vector(x + R_HEX * math.cos(math.radians(60 * v)), y,
                  z + R_HEX * math.sin(math.radians(60 * v)))
        for v in range(6)
    ]
    return cq.Wire.makePolygon(vs, close=True)


def circle_wire(r, x, z, y):
    return cq.Wire.makeCircle(r, cq.Vector(x, y, z), AXIS)


# ---------------- honeycomb cell centres (flat-top hexagons, columns along Z) -------
col_dx = PITCH * math.sqrt(3.0) / 2.0
cells = []
n = int(R_ARC / col_dx) + 2
m = int(R_ARC / PITCH) + 2
for i in range(-n, n + 1):
    x = i * col_dx
    for j in range(-m, m + 1):
        z = j * PITCH + (PITCH / 2.0 if i % 2 else 0.0)
        if i == 0 and j == 0:
            continue  # solid central land
        verts = [(x + R_HEX * math.cos(math.radians(60 * v)),
                  z + R_HEX * math.sin(math.radians(60 * v))) for v in range(6)]
        if all(inside_outline(v) and boundary_dist(v) >= EDGE_MARGIN for v in verts):
            cells.append((x, z))

Y1 = Y_FRONT               # front face
Y2 = Y_FRONT + D_CAV       # recess floor
Y3 = Y_FRONT + D_HEX       # bottom of the hex cells

# ---- layer 1: rim around the front recess, pierced by the hex cells ----
rim_cells = [c for c in cells if math.hypot(*c) - R_HEX > R_CAV]
cross_cells = [c for c in cells
               if math.hypot(*c) + R_HEX > R_CAV and math.hypot(*c) - R_HEX <= R_CAV]
f1 = cq.Face.makeFromWires(
    outline_wire(Y1),
    [circle_wire(R_CAV, 0, 0, Y1)] + [hex_wire(x, z, Y1) for x, z in rim_cells],
)
if cross_cells:
    cross = cq.Compound.makeCompound(
        [cq.Face.makeFromWires(hex_wire(x, z, Y1)) for x, z in cross_cells])
    f1 = f1.cut(cross)

# ---- layer 2: honeycomb floor of the recess (hex cells), solid central land ----
f2 = cq.Face.makeFromWires(outline_wire(Y2), [hex_wire(x, z, Y2) for x, z in cells])
land = cq.Face.makeFromWires(circle_wire(LAND_R, 0, 0, Y2))
f2 = f2.fuse(land)

# ---- layer 3: back skin with a round hole under every cell, same central land ----
f3 = cq.Face.makeFromWires(
    outline_wire(Y3),
    [circle_wire(HOLE_R, x, z, Y3) for x, z in cells],
)
f3 = f3.fuse(cq.Face.makeFromWires(circle_wire(LAND_R, 0, 0, Y3)))


def extrude_faces(f, d):
    return [cq.Solid.extrudeLinear(ff, cq.Vector(0, d, 0)) for ff in f.Faces()]


solids = (extrude_faces(f1, D_CAV) + extrude_faces(f2, D_HEX - D_CAV)
          + extrude_faces(f3, T - D_HEX))
body = solids[0].fuse(*solids[1:], glue=True).clean()

# small centre hole through the land
center_hole = cq.Solid.makeCylinder(CENTER_HOLE_D / 2.0, T + 2.0,
                                    cq.Vector(0, Y_FRONT - 1.0, 0), AXIS)
body = body.cut(center_hole)

result = cq.Workplane("XY").newObject([body])
VIEW = {"azimuth": 45, "elevation": 26}
